import cadquery as cq

# ---------------------------------------------------------------
# Pair of plain set-screw shaft collars lying flat on the XY plane,
# spaced along Y, each with one radial set-screw hole facing +X.
# All four circular edges of each collar are rounded.
# ---------------------------------------------------------------

# --- driving dimensions (mm) ---
OD = 25.0          # collar outer diameter
BORE = 10.0        # shaft bore diameter
WIDTH = 5.7        # collar axial width (along Z)
SET_D = 4.0        # radial set-screw hole diameter
SET_Z = WIDTH / 2  # height of the set-screw axis (mid-width)
PITCH = 33.5       # centre distance between neighbouring collars (along Y)
N_COLLARS = 2      # number of collars in the row
R_OUT = 0.6        # round on the outer (OD) edges, top and bottom
R_IN = 0.6         # round on the bore edges, top and bottom

VIEW = {"azimuth": 45, "elevation": 26}


def collar():
    ro, ri = OD / 2.0, BORE / 2.0
    # half cross-section in the (r, z) plane: rectangle with rounded corners
    prof = (
        cq.Sketch()
        .push([((ro + ri) / 2.0, WIDTH / 2.0)])
        .rect(ro - ri, WIDTH)
        .reset()
        .vertices(">X")
        .fillet(R_OUT)
        .reset()
        .vertices("<X")
        .fillet(R_IN)
    )
    # revolve the section a full turn about the global Z axis
    body = (
        cq.Workplane("XZ")
        .placeSketch(prof)
        .revolve(360.0, (0, 0, 0), (0, 1, 0))
    )
    # radial set-screw hole on +X, from the bore out through the wall
    hole_plane = cq.Plane(origin=(0, 0, SET_Z), xDir=(0, -1, 0), normal=(1, 0, 0))
    hole = cq.Workplane(hole_plane).circle(SET_D / 2.0).extrude(OD)
    return body.cut(hole)


c = collar()
y0 = -PITCH * (N_COLLARS - 1) / 2.0
result = c.translate((0, y0, 0))
for i in range(1, N_COLLARS):
    result = result.union(c.translate((0, y0 + i * PITCH, 0)))
